import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_O = 103.0        # outer radius of the big clamp arc (centre at origin)
T = 3.15           # strip thickness
H = 20.0           # strip width (height along Z)
LEG = 18.8         # straight leg below the arc centre line (before round end)
LOOP_RO = 26.6     # outer radius of the two small loops
LOOP_A = 40.0      # loop centre x offset (+/-); loops are tangent to big arc
LOOP_END = -55.0   # end angle of the left loop (deg, about loop centre)
U_DEPTH = 15.8     # U-channel floor below loop centres
U_FIL = 8.5        # fillet radius between U floor and loops
WEB_DROP = 18.6    # web underside (at centre) below loop centres

HOLE_D = 5.2       # end holes
HOLE_E = 8.0       # hole centre distance from the leg's straight end

PIN_S = 6.6        # square locating studs (side)
PIN_LEN = 6.5      # protrusion beyond outer face along the stud axis
PIN_FIL = 2.2      # rounding of the studs' long edges
PIN_END_FIL = 1.0  # rounding of the studs' end edges
# (position angle on big arc, stud axis direction) for the left side, degrees
PINS_LEFT = [(128.0, 82.0), (160.0, 205.0)]

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived geometry ----------------
R_I = R_O - T
LOOP_RI = LOOP_RO - T
LOOP_B = math.sqrt((R_O - LOOP_RO) ** 2 - LOOP_A ** 2)   # internal tangency
PHI = math.degrees(math.atan2(LOOP_B, -LOOP_A))        # tangent angle (left loop)
Y_U = LOOP_B - U_DEPTH
Y_WEB = LOOP_B - WEB_DROP


def pol(c, r, ang):
    a = math.radians(ang)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


def mx(p):
    return (-p[0], p[1])


def ang_of(c, p):
    return math.degrees(math.atan2(p[1] - c[1], p[0] - c[0]))


O = (0.0, 0.0)
CL = (-LOOP_A, LOOP_B)
CR = (LOOP_A, LOOP_B)

# --- U-channel fillet (left side) ---
dyf = Y_U + U_FIL - LOOP_B
xf = -LOOP_A + math.sqrt((LOOP_RO + U_FIL) ** 2 - dyf ** 2)
FU = (xf, Y_U + U_FIL)
BETA = ang_of(CL, FU)                      # tangent angle on loop outer circle
U_P1 = pol(CL, LOOP_RO, BETA)
U_P2 = (xf, Y_U)
U_MID = pol(FU, U_FIL, (ang_of(FU, U_P1) + 270.0) / 2.0)

# --- loop ends: full round cap at LOOP_END; web underside arc meets the cap ---
TIP_O = pol(CL, LOOP_RO, LOOP_END)                 # outer end point (left loop)
TIP_I = pol(CL, LOOP_RI, LOOP_END)                 # inner end point
_cc = pol(CL, (LOOP_RO + LOOP_RI) / 2.0, LOOP_END)
TIP_MID = (_cc[0] + (T / 2.0) * math.sin(math.radians(LOOP_END)),
           _cc[1] - (T / 2.0) * math.cos(math.radians(LOOP_END)))

phiR = 180.0 - PHI
rc = T / 2.0      # full round at the leg ends

# ---------------- profile (top view), one closed wire ----------------
w = cq.Workplane("XY").moveTo(-R_O, -LEG)
w = w.lineTo(-R_O, 0.0)
w = w.threePointArc(pol(O, R_O, (180.0 + PHI) / 2), pol(O, R_O, PHI))
w = w.threePointArc(pol(CL, LOOP_RO, (PHI + BETA) / 2), U_P1)
w = w.threePointArc(U_MID, U_P2)
w = w.lineTo(*mx(U_P2))
w = w.threePointArc(mx(U_MID), mx(U_P1))
w = w.threePointArc(pol(CR, LOOP_RO, (180.0 - BETA + phiR) / 2), pol(CR, LOOP_RO, phiR))
w = w.threePointArc(pol(O, R_O, phiR / 2), (R_O, 0.0))
w = w.lineTo(R_O, -LEG)
w = w.threePointArc((R_O - rc, -LEG - rc), (R_I, -LEG))
w = w.lineTo(R_I, 0.0)
w = w.threePointArc(pol(O, R_I, phiR / 2), pol(O, R_I, phiR))
w = w.threePointArc(pol(CR, LOOP_RI, (phiR + 180.0 - LOOP_END) / 2), mx(TIP_I))
w = w.threePointArc(mx(TIP_MID), mx(TIP_O))
w = w.threePointArc((0.0, Y_WEB), TIP_O)
w = w.threePointArc(TIP_MID, TIP_I)
w = w.threePointArc(pol(CL, LOOP_RI, (LOOP_END + PHI) / 2), pol(CL, LOOP_RI, PHI))
w = w.threePointArc(pol(O, R_I, (180.0 + PHI) / 2), (-R_I, 0.0))
w = w.lineTo(-R_I, -LEG)
w = w.threePointArc((-R_O + rc, -LEG - rc), (-R_O, -LEG))
w = w.close()

body = w.extrude(H)

# ---------------- end holes (one through-cylinder along X) ----------------
hole = cq.Workplane("XY").add(
    cq.Solid.makeCylinder(HOLE_D / 2, 2 * (R_O + 10.0),
                          cq.Vector(-(R_O + 10.0), -LEG + HOLE_E, H / 2), cq.Vector(1, 0, 0)))
body = body.cut(hole)


# ---------------- locating studs ----------------
def make_pin(pos_ang, dir_ang):
    bx, by = pol(O, R_O - T / 2, pos_ang)
    d = (math.cos(math.radians(dir_ang)), math.sin(math.radians(dir_ang)))
    bb = bx * d[0] + by * d[1]
    cc = bx * bx + by * by - R_O * R_O
    s_exit = -bb + math.sqrt(bb * bb - cc)
    back = 6.0
    length = back + s_exit + PIN_LEN
    pin = (
        cq.Workplane("XY")
        .box(length, PIN_S, PIN_S, centered=(False, True, False))
        .edges("|X")
        .fillet(PIN_FIL)
        .faces(">X")
        .edges()
        .fillet(PIN_END_FIL)
    )
    pin = pin.translate((-back, 0, 0)).rotate((0, 0, 0), (0, 0, 1), dir_ang).translate((bx, by, 0))
    return pin


pins = None
for pa, da in PINS_LEFT:
    for p in (make_pin(pa, da), make_pin(180.0 - pa, 180.0 - da)):
        pins = p if pins is None else pins.union(p)
# keep the studs outside the strip's inner face
inner = cq.Workplane("XY").circle(R_I + T / 2).extrude(H)
pins = pins.cut(inner)
body = body.union(pins)

result = body
